import cadquery as cq

# =====================================================================
# Mounting plate: chamfered plate with four side ears, two hinge lugs,
# a shallow divided tray underneath, vent patterns and end screw slots.
# Units: mm.  Plate underside at Z = 0, plate top at Z = T.
# =====================================================================

# ---------------- driving dimensions ----------------
W = 97.3          # plate width  (X)
L = 236.5         # plate length (Y)
T = 4.4           # plate thickness
R_CORNER = 12.0   # plate corner radius
CH_H = 3.8        # top edge chamfer, horizontal leg
CH_V = 2.2        # top edge chamfer, vertical leg

EAR_Y = 45.0      # ears at +/- EAR_Y on both long sides
EAR_OFF = 3.05    # ear centre outside the plate edge
EAR_R = 4.4       # ear radius
EAR_FIL = 4.5     # concave blend radius between ear and plate edge
EAR_HOLE = 3.4

BOX_W = 87.8      # open tray under the plate
BOX_L = 141.0
BOX_H = 9.8
BOX_R = 6.0
WALL = 2.0
DIV_T = 2.5       # divider wall thickness (crosses the centre hole)

LUG_X = 31.2      # hinge lugs standing on the top face
LUG_Y = -57.0
LUG_T = 4.3       # thickness along X
LUG_W = 8.8       # width along Y
LUG_H = 8.8       # height above the top face
LUG_HOLE = 4.8
LUG_HOLE_DEPTH = 2.5  # blind, from the outer face
LUG_FIL = 2.0

CENTER_HOLE = 10.5
PITCH = 5.65      # vent pattern: 45 deg grid, half-diagonal pitch
DIA_HOLE = 4.4
DIA_SMALL = 3.6
DIA_TIP = 46.2
DIA_SHIFT = 1.0   # both patterns sit slightly toward +Y

SLOT_Y = 93.5     # counterbored screw slots near the ends
SLOT_L, SLOT_W = 17.5, 6.3
SLOT_CB_L, SLOT_CB_W = 22.0, 10.8
CB_DEPTH = 2.0
SMALL_Y = 108.5   # counterbored holes at the very ends
SMALL_D, SMALL_CB = 5.5, 8.6

RECT_X = 29.0     # two rectangular windows
RECT_YS = (30.8, 14.5)
RECT_W, RECT_H = 7.3, 10.5

AUX_HOLE_Y = -57.0
AUX_HOLE_D = 6.0
AUX_BOSS_D, AUX_BOSS_H = 10.4, 5.8

BOSS_D, BOSS_HOLE, BOSS_H = 7.5, 2.5, 8.5     # PCB standoffs in the tray
BOSS_PTS = [(29.7, -47.9), (-22.4, -46.6), (29.7, 47.8), (-32.4, 46.0)]
RING_D, RING_H = 7.5, 1.5                     # short rings under the small vents


def xy(z=0.0):
    return cq.Workplane("XY").workplane(offset=z)


# ---------------- plate with ears ----------------
plate = xy().rect(W, L).extrude(T).edges("|Z").fillet(R_CORNER)

ear_pts = [(sx * (W / 2 + EAR_OFF), sy * EAR_Y) for sx in (-1, 1) for sy in (-1, 1)]
ears = xy().pushPoints(ear_pts).circle(EAR_R).extrude(T)
bridges = (xy().pushPoints([(x - (1 if x > 0 else -1) * EAR_OFF, y) for (x, y) in ear_pts])
           .rect(2 * EAR_OFF, 2 * EAR_R).extrude(T))
plate = plate.union(ears).union(bridges)


def _ear_junction(e):
    c = e.Center()
    for (x, y) in ear_pts:
        sx = 1 if x > 0 else -1
        if abs(c.x - sx * W / 2) < 0.6 and abs(abs(c.y - y) - EAR_R) < 0.6:
            return True
    return False


# concave blends between the ears and the straight plate edge
plate = plate.newObject([e for e in plate.edges("|Z").vals() if _ear_junction(e)]).fillet(EAR_FIL)

# chamfer around the whole top outline (runs over the ears as well)
outer = plate.faces(">Z").val().outerWire()
plate = plate.newObject(outer.Edges()).chamfer(CH_V, CH_H)

# ---------------- tray underneath ----------------
tray = xy(-BOX_H).rect(BOX_W, BOX_L).extrude(BOX_H).edges("|Z").fillet(BOX_R)
tray_in = (xy(-BOX_H).rect(BOX_W - 2 * WALL, BOX_L - 2 * WALL).extrude(BOX_H)
           .edges("|Z").fillet(BOX_R - WALL))
tray = tray.cut(tray_in)
divider = xy(-BOX_H).rect(BOX_W - 2 * WALL, DIV_T).extrude(BOX_H)

# standoffs, the boss under the auxiliary hole and the rings under the small vents
ring_pts = [(0, sgn * (DIA_TIP - 4 * PITCH) + DIA_SHIFT) for sgn in (1, -1)]
bosses = (xy(-BOSS_H).pushPoints(BOSS_PTS).circle(BOSS_D / 2).extrude(BOSS_H + 0.5)
          .union(xy(-AUX_BOSS_H).center(0, AUX_HOLE_Y).circle(AUX_BOSS_D / 2)
                 .extrude(AUX_BOSS_H + 0.5))
          .union(xy(-RING_H).pushPoints(ring_pts).circle(RING_D / 2).extrude(RING_H + 0.5)))

body = plate.union(tray).union(divider).union(bosses)

# ---------------- hinge lugs on the top face ----------------
for sx in (-1, 1):
    x = sx * LUG_X
    r = LUG_W / 2.0
    lug = (cq.Workplane("YZ", origin=(x - LUG_T / 2, 0, 0))
           .center(LUG_Y, T - 0.5)
           .moveTo(-r, 0).lineTo(-r, LUG_H + 0.5 - r)
           .threePointArc((0, LUG_H + 0.5), (r, LUG_H + 0.5 - r))
           .lineTo(r, 0).close()
           .extrude(LUG_T))
    lug = lug.edges(cq.selectors.BoxSelector((x - 10, LUG_Y - 10, T + 0.01),
                                             (x + 10, LUG_Y + 10, T + 20))).fillet(LUG_FIL)
    body = body.union(lug)

# blind pivot holes drilled into the outer face of each lug
lug_holes = None
for sx in (-1, 1):
    x_in = sx * (LUG_X + LUG_T / 2 - LUG_HOLE_DEPTH)   # bottom of the blind hole
    x_out = sx * (LUG_X + LUG_T / 2 + 1.0)             # just outside the lug
    h = (cq.Workplane("YZ", origin=(min(x_in, x_out), 0, 0))
         .center(LUG_Y, T + LUG_H - LUG_W / 2).circle(LUG_HOLE / 2)
         .extrude(abs(x_out - x_in)))
    lug_holes = h if lug_holes is None else lug_holes.union(h)

# ---------------- cutting tools ----------------
Z0 = -BOX_H - 1
HZ = BOX_H + T + 2

# vent patterns (45 deg grid, 13 holes each, one smaller hole)
vent_big, vent_small = [], []
for sgn in (1, -1):
    for u in range(4):
        for v in range(4):
            if (u, v) in ((3, 2), (2, 3), (3, 3)):
                continue
            p = ((u - v) * PITCH, sgn * (DIA_TIP - (u + v) * PITCH) + DIA_SHIFT)
            (vent_small if (u, v) == (2, 2) else vent_big).append(p)

cuts = (xy(-RING_H - 1).pushPoints(vent_big).circle(DIA_HOLE / 2).extrude(T + RING_H + 2)
        .union(xy(-RING_H - 1).pushPoints(vent_small).circle(DIA_SMALL / 2)
               .extrude(T + RING_H + 2))
        # auxiliary hole through its boss
        .union(xy(Z0).center(0, AUX_HOLE_Y).circle(AUX_HOLE_D / 2).extrude(HZ))
        # standoff bores (blind, from below)
        .union(xy(-BOSS_H - 1).pushPoints(BOSS_PTS).circle(BOSS_HOLE / 2).extrude(BOSS_H))
        # rectangular windows
        .union(xy(-1).pushPoints([(RECT_X, y) for y in RECT_YS])
               .rect(RECT_W, RECT_H).extrude(T + 2))
        # end slots / holes with counterbores
        .union(xy(-1).pushPoints([(0, SLOT_Y), (0, -SLOT_Y)])
               .slot2D(SLOT_L, SLOT_W, 0).extrude(T + 2))
        .union(xy(T - CB_DEPTH).pushPoints([(0, SLOT_Y), (0, -SLOT_Y)])
               .slot2D(SLOT_CB_L, SLOT_CB_W, 0).extrude(CB_DEPTH + 1))
        .union(xy(-1).pushPoints([(0, SMALL_Y), (0, -SMALL_Y)])
               .circle(SMALL_D / 2).extrude(T + 2))
        .union(xy(T - CB_DEPTH).pushPoints([(0, SMALL_Y), (0, -SMALL_Y)])
               .circle(SMALL_CB / 2).extrude(CB_DEPTH + 1))
        # ear holes
        .union(xy(-1).pushPoints(ear_pts).circle(EAR_HOLE / 2).extrude(T + 2))
        # lug cross holes
        .union(lug_holes)
        # centre hole through the plate only
        .union(xy().circle(CENTER_HOLE / 2).extrude(T + 1)))

body = body.cut(cuts)

# divider continues up through the centre hole as a round-topped bar
_br = DIV_T / 2.0
bar = (xy().rect(CENTER_HOLE + 1, DIV_T).extrude(T - _br)
       .union(cq.Workplane("YZ", origin=(-CENTER_HOLE / 2 - 0.5, 0, 0))
              .center(0, T - _br).circle(_br).extrude(CENTER_HOLE + 1))
       .intersect(xy().circle(CENTER_HOLE / 2 + 0.01).extrude(T)))
body = body.union(bar)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
